import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 63.6        # X size
L = 100.0       # Y size
H = 31.0        # Z size

STEP_X = 31.8   # step wall position (X)
STEP_Y = 62.5   # step +Y wall position
STEP_Z = 12.5   # step floor height

R_VERT = 3.75   # vertical corner radius
R_TOP = 3.5     # top edge fillet
R_STEP = 2.8    # step floor outer edge fillet
R_CONC = 3.2    # concave fillet at base of step +Y wall

HOLE_D = 6.0
CB_D = 12.0
CB_DEPTH = 8.0
HOLE_INSET_X = 9.2
HOLE_INSET_Y = 7.6

# windows through the step floor: (x0, x1, y0, y1)
WINDOWS = [
    (13.7, 30.0, 44.6, 57.3),
    (13.7, 30.0, 27.8, 40.4),
    (10.6, 31.2, 8.8, 21.3),
]
WIN_R = 0.6

EPS = 1e-3


class EdgeSel(cq.Selector):
    """select edges with a predicate on their bounding box"""

    def __init__(self, pred):
        self.pred = pred

    def filter(self, objs):
        out = []
        for o in objs:
            bb = o.BoundingBox()
            if self.pred(bb):
                out.append(o)
        return out


def near(a, b, tol=0.05):
    return abs(a - b) < tol


# ---------------- body ----------------
body = (
    cq.Workplane("XY")
    .box(W, L, H, centered=False)
    .edges("|Z")
    .fillet(R_VERT)
)

# step cut-out at (-X,-Y) corner
step = cq.Workplane("XY").box(STEP_X + 5, STEP_Y + 5, H, centered=False).translate((-5, -5, STEP_Z))
body = body.cut(step)

atZ = lambda e, z: near(e.zmin, z) and near(e.zmax, z)

# step floor outer edges (-X and -Y sides)
body = body.edges(EdgeSel(lambda e: atZ(e, STEP_Z) and (e.xmax < 0.01 or e.ymax < 0.01 or (e.xmax < R_VERT + 0.01 and e.ymax < R_VERT + 0.01)))).fillet(R_STEP)

# vertical convex edge at the -X end of the step's +Y wall
body = body.edges(EdgeSel(lambda e: near(e.xmin, 0) and near(e.xmax, 0) and near(e.ymin, STEP_Y) and near(e.ymax, STEP_Y))).fillet(R_VERT)

# concave fillet at base of the step's +Y wall
body = body.edges(EdgeSel(lambda e: atZ(e, STEP_Z) and near(e.ymin, STEP_Y, 1.5) and near(e.ymax, STEP_Y, 1.5) and e.xmax < STEP_X + EPS)).fillet(R_CONC)

# top edges (all edges on the top face except the sharp step-wall edge)
body = body.edges(EdgeSel(lambda e: atZ(e, H) and not (near(e.xmin, STEP_X) and near(e.xmax, STEP_X)))).fillet(R_TOP)

# rounded vertical corner where the step wall meets the -Y face (cut after the top fillet so the step-wall edge stays sharp)
R_SW = 3.0
corner = (
    cq.Workplane("XY")
    .box(R_SW + 1, R_SW + 1, H - STEP_Z + R_STEP + 1, centered=False)
    .translate((STEP_X - 1, -1, STEP_Z - R_STEP))
    .cut(cq.Workplane("XY").circle(R_SW).extrude(H + 2).translate((STEP_X + R_SW, R_SW, -1)))
)
body = body.cut(corner)

# ---------------- counterbored mounting holes ----------------
HOLES = [(HOLE_INSET_X, L - HOLE_INSET_Y), (W - HOLE_INSET_X, L - HOLE_INSET_Y), (W - HOLE_INSET_X, HOLE_INSET_Y)]
for (hx, hy) in HOLES:
    thru = cq.Workplane("XY").circle(HOLE_D / 2).extrude(H + 2).translate((hx, hy, -1))
    cb = cq.Workplane("XY").circle(CB_D / 2).extrude(CB_DEPTH + 1).translate((hx, hy, H - CB_DEPTH))
    body = body.cut(thru).cut(cb)

# ---------------- windows through the step floor ----------------
for (x0, x1, y0, y1) in WINDOWS:
    win = (
        cq.Workplane("XY")
        .rect(x1 - x0, y1 - y0)
        .extrude(STEP_Z + 2)
        .edges("|Z")
        .fillet(WIN_R)
        .translate(((x0 + x1) / 2, (y0 + y1) / 2, -1))
    )
    body = body.cut(win)

# ---------------- shallow recess in the bottom face ----------------
REC_RIM = 3.0
REC_D = 4.0
rec = (
    cq.Workplane("XY")
    .rect(W - 2 * REC_RIM, L - 2 * REC_RIM)
    .extrude(REC_D + 1)
    .edges("|Z")
    .fillet(max(R_VERT - REC_RIM, 0.5))
    .translate((W / 2, L / 2, -1))
)
body = body.cut(rec)

# ---------------- internal cavity behind the step wall ----------------
CAV_X0, CAV_X1 = 32.8, 51.0   # cavity X extent (open to the bottom recess)
CAV_Y0, CAV_Y1 = 13.8, STEP_Y # cavity Y extent (its +Y wall is flush with the step's +Y wall)
CAV_Z1 = 27.7                 # cavity ceiling (3.3 mm top skin)
OPEN_Y1 = STEP_Y              # the window in the step wall runs up to the step's +Y wall
OPEN_R = R_CONC               # rounding of the window's +Y corners (continues the concave fillet)
cav = cq.Workplane("XY").box(CAV_X1 - CAV_X0, CAV_Y1 - CAV_Y0, CAV_Z1 + 1, centered=False).translate((CAV_X0, CAV_Y0, -1))
opening = (
    cq.Workplane("YZ")
    .moveTo(CAV_Y0, STEP_Z)
    .lineTo(OPEN_Y1 - OPEN_R, STEP_Z)
    .radiusArc((OPEN_Y1, STEP_Z + OPEN_R), -OPEN_R)
    .lineTo(OPEN_Y1, CAV_Z1 - OPEN_R)
    .radiusArc((OPEN_Y1 - OPEN_R, CAV_Z1), -OPEN_R)
    .lineTo(CAV_Y0, CAV_Z1)
    .close()
    .extrude(CAV_X0 - STEP_X + 2)
    .translate((STEP_X - 1, 0, 0))
)
body = body.cut(cav).cut(opening)

# ---------------- cable entry channel at the +Y end ----------------
KH_XC = 31.9            # channel / round recess centre (X)
KH_SLOT_W = 18.0        # channel width
KH_Y0 = 66.5            # inner end of the channel
KH_CH_Z1 = 26.0         # ceiling of the channel
KH_RZ = 16.0            # centre height of the round recess in the end face
KH_R = 12.1             # radius of the round recess
KH_REC_D = 2.9          # depth of the round recess
GROOVE_R = 4.2          # vertical cable-tie grooves in the channel walls
GROOVE_Y = 74.2
kx0, kx1 = KH_XC - KH_SLOT_W / 2, KH_XC + KH_SLOT_W / 2
chan = cq.Workplane("XY").box(KH_SLOT_W, L - KH_Y0 + 1, KH_CH_Z1 + 1, centered=False).translate((kx0, KH_Y0, -1))
body = body.cut(chan)
kh_round = cq.Workplane("XZ").center(KH_XC, KH_RZ).circle(KH_R).extrude(-(KH_REC_D + 1)).translate((0, L - KH_REC_D, 0))
body = body.cut(kh_round)
for gx in (kx0, kx1):
    g = cq.Workplane("XY").circle(GROOVE_R).extrude(KH_CH_Z1 + 1).translate((gx, GROOVE_Y, -1))
    body = body.cut(g)

# ---------------- shallow grooves in the recess ceiling ----------------
GROOVE_DEPTH = 1.5
BOTTOM_GROOVES = [(6.3, 11.0, 30.9, 72.5), (52.75, 55.9, 30.7, 72.5)]
for (x0, x1, y0, y1) in BOTTOM_GROOVES:
    gv = cq.Workplane("XY").box(x1 - x0, y1 - y0, REC_D + GROOVE_DEPTH, centered=False).translate((x0, y0, 0))
    body = body.cut(gv)

# ---------------- counterbores on the underside of the mounting holes ----------------
CB_BOT_D = 11.5
for (hx, hy) in HOLES:
    cbb = cq.Workplane("XY").circle(CB_BOT_D / 2).extrude(REC_D + 1).translate((hx, hy, -1))
    body = body.cut(cbb)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
